import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_W = 100.0        # square base plate
PLATE_T = 4.35         # plate thickness
PLATE_CH = 9.0         # corner chamfer (vertical edges)

# main onion dome: profile (radius, height above plate top)
DOME_BASE_R = 30.4
DOME_CONE_SLOPE = 0.37     # dr/dh of the conical lower drum
DOME_CONE_H = 22.7         # height of the conical lower drum
DOME_TIP_H = 74.1
DOME_UPPER = [             # onion part above the drum
    (41.3, 36.5),
    (39.9, 44.1),
    (35.0, 52.3),
    (24.1, 60.5),
    (10.4, 67.7),
]

# main spire (heights above dome tip)
SPIRE_ROD_R = 0.5
SPIRE_LEN = 31.55
SPIRE_BALLS = [(1.65, 1.9), (4.1, 1.45), (SPIRE_LEN, 1.6), (SPIRE_LEN + 1.4, 0.8)]

# corner towers
TOWER_POS_R = 52.5     # distance of tower axis from centre
TOWER_ROT = 1.1        # small twist of the tower pattern (deg)
TOWER_R = 10.0         # drum radius
TOWER_H = 16.6         # drum height
BAND_IN_R = 10.35      # octagonal band inradius
BAND_H = 1.9
CAP_BASE_R = 10.75     # cap radius where it sits on the band
CAP_PROFILE = [        # (radius, height above plate top)
    (10.95, 20.5),
    (10.9, 22.2),
    (9.7, 24.2),
    (6.5, 26.4),
    (2.1, 28.85),
]
CAP_TIP = (0.5, 30.0)
CAP_T0 = (0.1, 1.0)    # start / end tangents of the cap profile
CAP_T1 = (-1.0, 0.45)
FIN_ROD_R = 0.5
FIN_BALL_R = 1.0
FIN_BALL_H = 36.6

# pointed windows (6 per tower, shallow pockets)
WIN_N = 6
WIN_W = 5.2
WIN_BOT = 1.5
WIN_SHOULDER = 4.7
WIN_PEAK = 6.7
WIN_DEPTH = 5.0

SEAM_DIR = 135.0       # main dome revolve seam on the back side (towers: facing the dome)

T = PLATE_T


def revolve_profile(r0, z0, pts, tip, t0, t1):
    """Closed half-profile in XZ from the axis, revolved about Z."""
    wp = (
        cq.Workplane("XZ")
        .moveTo(0, z0)
        .lineTo(r0, z0)
        .spline(pts + [tip], tangents=[t0, t1], includeCurrent=True)
    )
    if tip[0] > 1e-6:
        wp = wp.lineTo(0, tip[1])
    return wp.close().revolve(360, (0, 0, 0), (0, 1, 0))


# ---------------- base plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(PLATE_W, PLATE_W)
    .extrude(T)
    .edges("|Z")
    .chamfer(PLATE_CH)
)

# ---------------- main dome ----------------
cone_pts = [
    (DOME_BASE_R + DOME_CONE_SLOPE * DOME_CONE_H * f, DOME_CONE_H * f) for f in (0.5, 1.0)
]
dome = revolve_profile(
    DOME_BASE_R, T,
    [(r, T + h) for r, h in cone_pts + DOME_UPPER],
    (0.0, T + DOME_TIP_H),
    (DOME_CONE_SLOPE, 1.0), (-1.0, 0.65),
).rotate((0, 0, 0), (0, 0, 1), SEAM_DIR)

# ---------------- main spire ----------------
zt = T + DOME_TIP_H
spire = (
    cq.Workplane("XY")
    .workplane(offset=zt - 1.0)
    .circle(SPIRE_ROD_R)
    .extrude(SPIRE_LEN + 1.0)
)
for zc, rb in SPIRE_BALLS:
    spire = spire.union(cq.Workplane("XY").sphere(rb).translate((0, 0, zt + zc)))
spire = spire.rotate((0, 0, 0), (0, 0, 1), SEAM_DIR)

main = plate.union(dome).union(spire)


# ---------------- one corner tower (built on its own axis) ----------------
def make_tower(rot, seam_dir):
    """Tower whose window/band pattern is turned by `rot` deg; revolve seams at `seam_dir`."""
    seam = seam_dir - rot
    drum = (
        cq.Workplane("XY").workplane(offset=T).circle(TOWER_R).extrude(TOWER_H)
        .rotate((0, 0, 0), (0, 0, 1), seam)
    )
    band = (
        cq.Workplane("XY")
        .workplane(offset=T + TOWER_H)
        .transformed(rotate=(0, 0, 22.5))
        .polygon(8, 2 * BAND_IN_R / math.cos(math.radians(22.5)))
        .extrude(BAND_H)
    )
    hb = TOWER_H + BAND_H
    cap = revolve_profile(
        CAP_BASE_R, T + hb,
        [(r, T + h) for r, h in CAP_PROFILE],
        (CAP_TIP[0], T + CAP_TIP[1]),
        CAP_T0, CAP_T1,
    ).rotate((0, 0, 0), (0, 0, 1), seam)
    fin = (
        cq.Workplane("XY")
        .workplane(offset=T + CAP_TIP[1] - 0.5)
        .circle(FIN_ROD_R)
        .extrude(FIN_BALL_H - CAP_TIP[1] + 0.5)
        .rotate((0, 0, 0), (0, 0, 1), seam)
    )
    ball = (
        cq.Workplane("XY").sphere(FIN_BALL_R)
        .rotate((0, 0, 0), (0, 0, 1), seam)
        .translate((0, 0, T + FIN_BALL_H))
    )
    tw = drum.union(band).union(cap).union(fin).union(ball)

    half = WIN_W / 2.0
    win_pts = [
        (-half, WIN_BOT),
        (half, WIN_BOT),
        (half, WIN_SHOULDER),
        (0.0, WIN_PEAK),
        (-half, WIN_SHOULDER),
    ]
    for k in range(WIN_N):
        cutter = (
            cq.Workplane("YZ")
            .workplane(offset=TOWER_R - WIN_DEPTH)
            .polyline([(x, T + z) for x, z in win_pts])
            .close()
            .extrude(WIN_DEPTH + 2.0)
            .rotate((0, 0, 0), (0, 0, 1), 360.0 / WIN_N * k)
        )
        tw = tw.cut(cutter)
    return tw.rotate((0, 0, 0), (0, 0, 1), rot)


# the (+x,-y) tower has windows at 0,60,..deg; the others are 90 deg copies
result = main
for k in range(4):
    rot = 90.0 * k + TOWER_ROT
    a_deg = -45.0 + rot
    a = math.radians(a_deg)
    t = make_tower(rot, a_deg + 180.0).translate((TOWER_POS_R * math.cos(a), TOWER_POS_R * math.sin(a), 0))
    result = result.union(t)

VIEW = {"azimuth": 45, "elevation": 26}
